import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BX = 100.0          # block size along X
BY = 98.0           # block size along Y
BH = 37.0           # block height
# vertical corner radii of the upper part: (+X+Y, -X+Y, -X-Y, +X-Y)
RC_UP = (12.5, 12.5, 14.0, 12.5)
RC_STEP = 1.3       # lower part corners are rounded this much more (small ledge)
SEAM_Z = 22.6       # height of the upper/lower split above block bottom

PL = 239.0          # plate length (along Y)
PH = 31.2           # plate height
P_DROP = 5.8        # plate top below block top
P_YOFF = 2.8        # plates centre offset in +Y relative to block centre
# plates as (x_min, x_max) relative to block centre
PLATES = [(-36.8, -28.6), (-22.8, -14.6), (11.3, 19.5), (27.1, 36.8)]
END_SEG = 53.0      # length of the separate end pieces of every plate
HOLE_D = 6.6        # cross hole diameter in the end pieces
HOLE_END = 9.6      # hole centre distance from plate end

CYL_D = 79.0        # body cylinder diameter
CYL_H = 82.0        # body cylinder height (below block)
CYL_X = -2.1        # cylinder axis offset from block centre
CYL_Y = -2.7

WIRE_D = 4.4        # helical bead diameter
WIRE_OUT = 4.2      # bead protrusion beyond the cylinder surface
HELIX_START = 0.0   # deg, angle where the bead starts at the cylinder bottom
HELIX_SPAN = 326.6  # deg, angle over which the bead rises one cylinder height

# z = 0 at the block bottom; cylinder hangs below
# ---------------- block (two stacked rounded slabs) ----------------
def rounded_rect(wp, w, h, radii):
    """closed outline of a w x h rectangle centred on the origin with per-corner radii
    (order: +X+Y, -X+Y, -X-Y, +X-Y)"""
    hx, hy = w / 2.0, h / 2.0
    r1, r2, r3, r4 = radii
    c = math.cos(math.radians(45.0))
    wp = wp.moveTo(hx, -hy + r4).lineTo(hx, hy - r1)
    wp = wp.threePointArc((hx - r1 + r1 * c, hy - r1 + r1 * c), (hx - r1, hy))
    wp = wp.lineTo(-hx + r2, hy)
    wp = wp.threePointArc((-hx + r2 - r2 * c, hy - r2 + r2 * c), (-hx, hy - r2))
    wp = wp.lineTo(-hx, -hy + r3)
    wp = wp.threePointArc((-hx + r3 - r3 * c, -hy + r3 - r3 * c), (-hx + r3, -hy))
    wp = wp.lineTo(hx - r4, -hy)
    wp = wp.threePointArc((hx - r4 + r4 * c, -hy + r4 - r4 * c), (hx, -hy + r4))
    return wp.close()


lower = rounded_rect(cq.Workplane("XY"), BX, BY, [r + RC_STEP for r in RC_UP]).extrude(SEAM_Z)
upper = rounded_rect(cq.Workplane("XY").workplane(offset=SEAM_Z), BX, BY, RC_UP).extrude(BH - SEAM_Z)
block = lower.union(upper)

# ---------------- plates ----------------
z_pb = BH - P_DROP - PH          # plate bottom
z_pc = z_pb + PH / 2.0           # plate mid height


def plate(x0, x1):
    t = x1 - x0
    xc = (x0 + x1) / 2.0
    bar = (
        cq.Workplane("XY")
        .box(t, PL, PH, centered=(True, True, False))
        .translate((xc, P_YOFF, z_pb))
    )
    for s in (-1, 1):
        yh = P_YOFF + s * (PL / 2.0 - HOLE_END)
        hole = (
            cq.Workplane("YZ")
            .workplane(offset=x0 - 1.0)
            .center(yh, z_pc)
            .circle(HOLE_D / 2.0)
            .extrude(t + 2.0)
        )
        bar = bar.cut(hole)
    return bar


plates = None
for (x0, x1) in PLATES:
    p = plate(x0, x1)
    plates = p if plates is None else plates.union(p)

# ---------------- cylinder ----------------
R = CYL_D / 2.0
cyl = (
    cq.Workplane("XY")
    .circle(R)
    .extrude(CYL_H + 1.0)
    .rotate((0, 0, 0), (0, 0, 1), 180)   # keep the surface seam on the -X side
    .translate((CYL_X, CYL_Y, -CYL_H))
)

# ---------------- helical bead ----------------
r = WIRE_D / 2.0
rh = R + WIRE_OUT - r                       # radius of the bead centre line
pitch = CYL_H * 360.0 / HELIX_SPAN
extra = 25.0                                # deg run-on into the block
hel_h = (HELIX_SPAN + extra) / 360.0 * pitch
helix = cq.Wire.makeHelix(pitch, hel_h, rh)
helix = helix.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), HELIX_START).translate(
    cq.Vector(CYL_X, CYL_Y, -CYL_H)
)
p0 = helix.startPoint()
tan0 = helix.tangentAt(0)
prof = cq.Wire.makeCircle(r, p0, tan0)
bead = cq.Solid.sweep(prof, [], helix, isFrenet=True)
bead = cq.Workplane("XY").add(bead)
trim = (
    cq.Workplane("XY")
    .workplane(offset=-CYL_H)
    .center(CYL_X, CYL_Y)
    .rect(CYL_D + 20, CYL_D + 20)
    .extrude(CYL_H + BH * 0.5)
)
bead = bead.intersect(trim)

body = cyl.union(bead)
solid = block.union(body).union(plates).val()

# ---------------- joint lines of the bolted-on end pieces ----------------
# every plate is an inner bar with a separate end piece at each end; the joints
# show as lines across the top and bottom faces (imprinted, no volume change)
joint_edges = []
for (x0, x1) in PLATES:
    for s in (-1, 1):
        yj = P_YOFF + s * (PL / 2.0 - END_SEG)
        for zf in (z_pb, z_pb + PH):
            joint_edges.append(cq.Edge.makeLine(cq.Vector(x0, yj, zf), cq.Vector(x1, yj, zf)))
imprinted = solid.split(*joint_edges).Solids()
if len(imprinted) == 1 and imprinted[0].isValid():
    solid = imprinted[0]

result = cq.Workplane("XY").add(solid)

VIEW = {"azimuth": 45, "elevation": 26}
